import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 26.5          # overall width (X)
t_wall = 0.85     # side wall thickness (lower part)
t_lip = 2.05      # side wall thickness at the top lip / frame border
h_lip = 4.45      # depth of the top lip below the top surface
h_notch = 2.5     # height of the notches in the lip
notch_s = [(32.1, 39.8), (43.3, 50.9)]   # notches along each arm (arm coord.)
notch_c = (1.7, 9.3)                     # notches in the centre section (|Y|)
t_pocket = 0.2    # remaining wall behind the notches
a = 16.5          # half length of the flat top between the bends
Zt = 21.45        # height of the flat top
ANG = 30.0        # arm inclination (deg)
Zv = -1.2         # virtual apex of the V underside (lowest point is Z=0)
r_bend = 5.0      # round at the top bends
s_end = 58.36     # extent of the arm ends, measured along the arm
hole_d = 4.9      # pivot hole diameter
Z_hole = 5.9      # pivot hole height

cap_s0 = -3.33    # end cap ellipse centre (along arm, from the arm end)
cap_A = 5.82      # end cap ellipse major semi-axis
cap_th = -75.0    # end cap ellipse axis tilt relative to the arm (deg)

Y_bb_in = 11.3    # bend cross bars: inner (centre side) limit
Y_bb_out = 21.5   # bend cross bars: outer (arm window side) limit
Z_bb_bot = 16.6   # bend cross bars: underside height
r_bb = 2.0        # round on the outer lower edge of the bend bars
A_keel = 6.7      # keel (bottom cross bar): elliptic section half width
Z_keel_top = 10.5 # keel top height (ellipse is tangent to the underside)
s_bar_top = 53.3  # end bar inner face, arm coordinate at the top surface
s_bar_bot = 54.8  # end bar inner face, arm coordinate at the underside

VIEW = {"azimuth": 45, "elevation": 26}

ca = math.cos(math.radians(ANG))
sa = math.sin(math.radians(ANG))
ta = math.tan(math.radians(ANG))

# arm frame (+Y arm): s along the arm, p normal to it (up)
p_top = (Zt - a * ta) * ca          # top line offset
p_bot = Zv * ca                     # underside line offset
T = p_top - p_bot                   # arm thickness


def arm_pt(s, p, side=1):
    """(s,p) in the +Y arm frame -> (Y,Z); side=-1 mirrors to the -Y arm"""
    y = s * ca - p * sa
    z = s * sa + p * ca
    return (side * y, z)


def V(p):
    return cq.Vector(0.0, p[0], p[1])


def prism(pts2d, x0, x1):
    """closed (Y,Z) polygon extruded from X=x0 to X=x1"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts2d).close()
            .extrude(x1 - x0))


def rod(yc, zc, r, x0, x1):
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(yc, zc).circle(r)
            .extrude(x1 - x0))


def fillet(Vx, A, B, r):
    ux, uy = A[0] - Vx[0], A[1] - Vx[1]
    n = math.hypot(ux, uy)
    u1 = (ux / n, uy / n)
    ux, uy = B[0] - Vx[0], B[1] - Vx[1]
    n = math.hypot(ux, uy)
    u2 = (ux / n, uy / n)
    th = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
    d = r / math.tan(th / 2)
    bx, by = u1[0] + u2[0], u1[1] + u2[1]
    n = math.hypot(bx, by)
    bis = (bx / n, by / n)
    k = r / math.sin(th / 2) - r
    return ((Vx[0] + u1[0] * d, Vx[1] + u1[1] * d),
            (Vx[0] + bis[0] * k, Vx[1] + bis[1] * k),
            (Vx[0] + u2[0] * d, Vx[1] + u2[1] * d))


# ---------------- side profile (Y,Z) ----------------
# end cap: one tilted elliptical arc tangent to the top and underside lines
hT = T / 2
p_mid = (p_top + p_bot) / 2
thc = math.radians(cap_th)
cap_B = math.sqrt((hT ** 2 - (cap_A * math.sin(thc)) ** 2) / math.cos(thc) ** 2)


def cap_sp(t):
    x, y = cap_A * math.cos(t), cap_B * math.sin(t)
    return (s_end + cap_s0 + x * math.cos(thc) - y * math.sin(thc),
            p_mid + x * math.sin(thc) + y * math.cos(thc))


t_bot = math.atan2(cap_B * math.cos(thc), cap_A * math.sin(thc))  # p extreme
if cap_sp(t_bot)[1] > p_mid:
    t_bot += math.pi
t_top = t_bot + math.pi
capR = [arm_pt(*cap_sp(t_bot), 1), arm_pt(*cap_sp(t_top), 1)]
capL = [(-y, z) for y, z in capR]
cen = arm_pt(s_end + cap_s0, p_mid, 1)
xdir = (math.cos(thc) * ca - math.sin(thc) * sa, math.cos(thc) * sa + math.sin(thc) * ca)
cap_edge = cq.Edge.makeEllipse(
    cap_A, cap_B, cq.Vector(0, *cen), cq.Vector(1, 0, 0), cq.Vector(0, *xdir),
    math.degrees(t_bot), math.degrees(t_top), 1)

# keel ellipse: half width A_keel, top at Z_keel_top, tangent to the
# underside lines; its lower arc also forms the rounded bottom of the V
mk = ta
B_keel = ((Zv - Z_keel_top) ** 2 - (A_keel * mk) ** 2) / (2 * (Z_keel_top - Zv))
Zc_keel = Z_keel_top - B_keel
yk = A_keel ** 2 * mk / math.sqrt((A_keel * mk) ** 2 + B_keel ** 2)
zk = Zv + mk * yk
tk = math.degrees(math.atan2((zk - Zc_keel) / B_keel, yk / A_keel))
fa = ((-yk, zk), None, (yk, zk))
apex_edge = cq.Edge.makeEllipse(
    A_keel, B_keel, cq.Vector(0, 0, Zc_keel), cq.Vector(1, 0, 0),
    cq.Vector(0, 1, 0), 180 - tk, 360 + tk, 1)

bend_R = (a, Zt)
bend_L = (-a, Zt)
fbR = fillet(bend_R, capR[-1], bend_L, r_bend)
fbL = fillet(bend_L, bend_R, capL[-1], r_bend)

edges = [
    cq.Edge.makeLine(V(fa[2]), V(capR[0])),
    cap_edge,
    cq.Edge.makeLine(V(capR[-1]), V(fbR[0])),
    cq.Edge.makeThreePointArc(V(fbR[0]), V(fbR[1]), V(fbR[2])),
    cq.Edge.makeLine(V(fbR[2]), V(fbL[0])),
    cq.Edge.makeThreePointArc(V(fbL[0]), V(fbL[1]), V(fbL[2])),
    cq.Edge.makeLine(V(fbL[2]), V(capL[-1])),
    cap_edge.mirror("XZ"),
    cq.Edge.makeLine(V(capL[0]), V(fa[0])),
    apex_edge,
]
wire = cq.Wire.assembleEdges(edges)
face = cq.Face.makeFromWires(wire).translate(cq.Vector(-W / 2, 0, 0))
outer = cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(W, 0, 0)))

# ---------------- internal cavity ----------------
xi = W / 2 - t_wall            # inner face of the thin walls
slab = cq.Workplane("XY").box(2 * xi, 200, 200)


def end_bar(side):
    q1 = arm_pt(s_bar_top, p_top, side)
    q0 = arm_pt(s_bar_bot, p_bot, side)
    d = (q1[0] - q0[0], q1[1] - q0[1])
    n = math.hypot(*d)
    d = (d[0] / n, d[1] / n)
    qa = (q0[0] - 10 * d[0], q0[1] - 10 * d[1])
    qb = (q0[0] + 25 * d[0], q0[1] + 25 * d[1])
    qc = (qb[0] + side * 30, qb[1])
    qd = (qa[0] + side * 30, qa[1])
    return prism([qa, qb, qc, qd], -xi, xi)


bars = end_bar(1).union(end_bar(-1))

# bars under the top bends: flat outer face, rounded underside
Rq = Zt - Z_bb_bot
bb = (
    cq.Workplane("YZ", origin=(-xi, 0, 0))
    .moveTo(Y_bb_in, Zt + 15)
    .lineTo(Y_bb_in, Zt)
    .threePointArc((Y_bb_in + Rq * (1 - math.sqrt(0.5)), Zt - Rq * math.sqrt(0.5)),
                   (Y_bb_in + Rq, Z_bb_bot))
    .lineTo(Y_bb_out - r_bb, Z_bb_bot)
    .threePointArc((Y_bb_out - r_bb * (1 - math.sqrt(0.5)), Z_bb_bot + r_bb * (1 - math.sqrt(0.5))),
                   (Y_bb_out, Z_bb_bot + r_bb))
    .lineTo(Y_bb_out, Zt + 15)
    .close()
    .extrude(2 * xi)
)
bars = bars.union(bb).union(bb.mirror("XZ"))

# keel at the bottom of the V
keel = (cq.Workplane("YZ", origin=(-xi, 0, 0)).center(0, Zc_keel)
        .ellipse(A_keel - 0.05, B_keel - 0.05).extrude(2 * xi))
bars = bars.union(keel)

# top lips along the inner top edge of both side walls
yb = a + h_lip * math.tan(math.radians(ANG / 2))
far = 70.0
lo = [(-far, Zt + ta * (far - a) - h_lip / ca), (-yb, Zt - h_lip),
      (yb, Zt - h_lip), (far, Zt + ta * (far - a) - h_lip / ca)]
band = lo + [(p[0], p[1] + 40) for p in reversed(lo)]
xl = W / 2 - t_lip
bars = bars.union(prism(band, xl, xi)).union(prism(band, -xi, -xl))

cavity = slab.cut(bars)
body = outer.cut(cavity)

# ---------------- pockets in the lips (two per arm, two in the centre) ----
p_lb = p_top - h_lip                      # lip underside in the arm frame
pk0 = -0.15                               # pockets start just below the lip
pockets = []
for sy in (1, -1):
    for s1, s2 in notch_s:
        pockets.append([arm_pt(s1, p_lb + pk0, sy), arm_pt(s2, p_lb + pk0, sy),
                        arm_pt(s2, p_lb + h_notch, sy),
                        arm_pt(s1, p_lb + h_notch, sy)])
    y1, y2 = notch_c
    z0, z1 = Zt - h_lip + pk0, Zt - h_lip + h_notch
    pockets.append([(sy * y1, z0), (sy * y2, z0), (sy * y2, z1), (sy * y1, z1)])
xf = W / 2 - t_pocket
for poly in pockets:
    body = body.cut(prism(poly, xl - 0.5, xf)).cut(prism(poly, -xf, -xl + 0.5))

# ---------------- pivot hole ----------------
body = body.cut(rod(0, Z_hole, hole_d / 2, -W, W))

result = body
